import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
W = 170.0          # plate width (X)
T = 5.6            # sheet thickness

A1 = 15.0          # slope of lower (front) section, deg
A2 = 30.0          # slope of middle (window) section, deg
A3 = 0.0           # slope of rear lip, deg

L1 = 159.4         # lower section length along slope (top surface, sharp corners)
L2 = 77.5          # middle section length along slope
L3 = 14.7          # rear lip length

FRONT_UNDERCUT = 4.2   # bottom face of the front end set back (slanted end face)
LIP_UNDERCUT = 3.4     # bottom face of the lip end set forward (slanted end face)

R_FRONT = 10.0     # plan radius of front corners
R_BACK = 2.0       # plan radius of rear corners

# recess (pocket) in the lower section
REC_W = 133.5
REC_V0 = 6.3       # start along slope from front edge
REC_V1 = 155.0     # end along slope
REC_D = 1.5        # pocket depth

# slot in the lower section
SLOT_W = 48.0
SLOT_V0 = 11.6
SLOT_V1 = 25.0

# window in the middle section
WIN_W = 137.6
WIN_V0 = 15.5      # along slope from bend-1 corner
WIN_V1 = 63.5

# counterbored holes
HOLE_X = 71.6
HOLE_D = 6.4
CB_D = 11.0
CB_DEPTH = 1.2
H_FRONT_V = 13.4   # lower section, from front edge
H_MID_V = 9.6      # middle section, from bend-1 corner
H_TOP_V = 69.0     # middle section, from bend-1 corner


# ---------------- profile (Y,Z) ----------------
def dirv(a):
    r = math.radians(a)
    return (math.cos(r), math.sin(r))


def nrm(a):
    r = math.radians(a)
    return (-math.sin(r), math.cos(r))


def add(p, q, k=1.0):
    return (p[0] + k * q[0], p[1] + k * q[1])


def line_isect(p, d, q, e):
    # p + s d = q + u e
    det = d[0] * (-e[1]) - d[1] * (-e[0])
    rx, ry = q[0] - p[0], q[1] - p[1]
    s = (rx * (-e[1]) - ry * (-e[0])) / det
    return (p[0] + s * d[0], p[1] + s * d[1])


d1, d2, d3 = dirv(A1), dirv(A2), dirv(A3)
n1, n2, n3 = nrm(A1), nrm(A2), nrm(A3)

P0 = (0.0, 0.0)
P1 = add(P0, d1, L1)
P2 = add(P1, d2, L2)
P3 = add(P2, d3, L3)

Q0 = add(P0, n1, -T)
Q1 = line_isect(add(P0, n1, -T), d1, add(P1, n2, -T), d2)
Q2 = line_isect(add(P1, n2, -T), d2, add(P2, n3, -T), d3)
Q3 = add(P3, n3, -T)

Q0 = add(Q0, d1, FRONT_UNDERCUT)
Q3 = add(Q3, d3, -LIP_UNDERCUT)

# sharp bends, constant thickness (mitred corners)
prof = cq.Workplane("YZ").polyline([P0, P1, P2, P3, Q3, Q2, Q1, Q0]).close()
body = prof.extrude(W / 2.0, both=True)


# ---------------- section work planes ----------------
def sec_plane(origin_yz, ang):
    r = math.radians(ang)
    return cq.Plane(
        origin=(0.0, origin_yz[0], origin_yz[1]),
        xDir=(1.0, 0.0, 0.0),
        normal=(0.0, -math.sin(r), math.cos(r)),
    )


pl1 = sec_plane(P0, A1)
pl2 = sec_plane(P1, A2)


# ---------------- plan corner rounding ----------------
# plan-view outline with rounded corners, cut vertically (Z) through the bent plate
def corner_cutter(yc, sy, sx, R):
    """yc: Y of the edge at the corner; sy: +1 if the plate lies toward +Y."""
    e = 2.0
    xe = W / 2.0
    z0, z1 = -T - 20.0, 100.0
    pts = [
        (sx * (xe + e), yc - sy * e),
        (sx * (xe - R), yc - sy * e),
        (sx * (xe - R), yc),
    ]
    c = (sx * (xe - R), yc + sy * R)
    mid = (c[0] + sx * R * math.cos(math.radians(45)), c[1] - sy * R * math.sin(math.radians(45)))
    end = (sx * xe, yc + sy * R)
    wp = (
        cq.Workplane("XY", origin=(0, 0, z0))
        .moveTo(*pts[0])
        .lineTo(*pts[1])
        .lineTo(*pts[2])
        .threePointArc(mid, end)
        .lineTo(sx * (xe + e), yc + sy * R)
        .close()
        .extrude(z1 - z0)
    )
    return wp


for sx in (-1, 1):
    body = body.cut(corner_cutter(P0[0], 1, sx, R_FRONT))
    body = body.cut(corner_cutter(P3[0], -1, sx, R_BACK))


# recess pocket on lower section
rec = (
    cq.Workplane(pl1)
    .workplane(offset=1.0)
    .center(0, (REC_V0 + REC_V1) / 2.0)
    .rect(REC_W, REC_V1 - REC_V0)
    .extrude(-(1.0 + REC_D))
)
body = body.cut(rec)

# slot through lower section
slot = (
    cq.Workplane(pl1)
    .workplane(offset=1.0)
    .center(0, (SLOT_V0 + SLOT_V1) / 2.0)
    .rect(SLOT_W, SLOT_V1 - SLOT_V0)
    .extrude(-(T + 3.0))
)
body = body.cut(slot)

# window through middle section
win = (
    cq.Workplane(pl2)
    .workplane(offset=1.0)
    .center(0, (WIN_V0 + WIN_V1) / 2.0)
    .rect(WIN_W, WIN_V1 - WIN_V0)
    .extrude(-(T + 3.0))
)
body = body.cut(win)


# counterbored holes
def cb_holes(pl, pts):
    bore = cq.Workplane(pl).workplane(offset=1.0).pushPoints(pts).circle(HOLE_D / 2.0).extrude(-(T + 3.0))
    cb = cq.Workplane(pl).workplane(offset=1.0).pushPoints(pts).circle(CB_D / 2.0).extrude(-(1.0 + CB_DEPTH))
    return bore.union(cb)


body = body.cut(cb_holes(pl1, [(-HOLE_X, H_FRONT_V), (HOLE_X, H_FRONT_V)]))
body = body.cut(cb_holes(pl2, [(-HOLE_X, H_MID_V), (HOLE_X, H_MID_V),
                               (-HOLE_X, H_TOP_V), (HOLE_X, H_TOP_V)]))

result = body
